import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 600.0          # length along X
W = 310.0          # width along Y
H = 230.0          # height along Z

RIDGE_X = 88.0     # where the flat top starts sloping down toward +X
SLOPE_DROP = 47.0  # drop of the sloped top at the +X end

NX_CH_V = 73.0     # -X bottom chamfer (vertical, horizontal)
NX_CH_H = 49.0
PX_CH_V = 45.0     # +X bottom chamfer
PX_CH_H = 28.0

# axle bosses on the long sides
BOSS_X = (-176.0, 199.0)
BOSS_Z = 41.0
BOSS_D = 44.0
BOSS_OUT = 30.0
BOSS_BORE = 30.0

# end handles
HANDLE_ROD = 11.0
HANDLE_SPAN = 152.0
HANDLE_OUT = 33.0
HANDLE_R = 12.0
HANDLE_Z_NEG = 82.0
HANDLE_Z_POS = 50.0

# hood / chute on the sloped top
HOOD_W = 82.0
HOOD_T = 3.0
HOOD_TIP_X = 297.0
HOOD_TIP_RISE = 16.0
HOOD_BACK_X = 218.0   # vertical back wall of the chute
HOOD_END_X = 254.0    # where the side walls leave the slope
WELL_END_X = 295.0    # end of the opening in the slope
WELL_FLOOR_Z = 125.0

# fan grille on the slope
FAN_X = 219.0
FAN_Y = 98.0
FAN_D = 66.0

# ---------------- helpers ----------------
SLOPE_ANG = math.atan2(SLOPE_DROP, L / 2 - RIDGE_X)


def z_slope(x):
    """top surface height at position x"""
    if x <= RIDGE_X:
        return H
    return H - (x - RIDGE_X) * math.tan(SLOPE_ANG)


def mkplane(origin, xdir, ydir):
    """plane from origin, local x and local y directions"""
    xv = cq.Vector(xdir)
    yv = cq.Vector(ydir)
    return cq.Plane(origin=origin, xDir=xv, normal=xv.cross(yv))


def slope_wp(x, y):
    """workplane lying on the sloped top, local y = world +Y"""
    xd = (math.cos(SLOPE_ANG), 0.0, -math.sin(SLOPE_ANG))
    return cq.Workplane(mkplane((x, y, z_slope(x)), xd, (0, 1, 0)))


def face_wp(axis, sign, offset=0.0):
    """workplane on an outer side face, normal pointing outward, local y = world Z.
    use fpt() to convert world (horizontal, z) to local coordinates"""
    if axis == "x":
        org = (sign * (L / 2 + offset), 0, 0)
        xd = (0, 1, 0) if sign > 0 else (0, -1, 0)
    else:
        org = (0, sign * (W / 2 + offset), 0)
        xd = (1, 0, 0) if sign < 0 else (-1, 0, 0)
    return cq.Workplane(mkplane(org, xd, (0, 0, 1)))


def fpt(axis, sign, h, z):
    flip = (axis == "x" and sign > 0) or (axis == "y" and sign < 0)
    return (h if flip else -h, z)


def xz_prism(pts, y0, y1):
    """prism from an XZ polygon, spanning y0..y1"""
    wp = cq.Workplane(mkplane((0, y1, 0), (1, 0, 0), (0, 0, 1)))
    return wp.polyline(pts).close().extrude(y1 - y0)


def cyl(r, p0, d, length):
    return cq.Workplane(obj=cq.Solid.makeCylinder(r, length, cq.Vector(p0), cq.Vector(d)))


def handle(x_face, direction, z):
    """U shaped round-bar handle standing out of an X end face"""
    r = HANDLE_ROD / 2.0
    x0 = x_face - direction * 6.0          # legs start inside the wall
    xo = x_face + direction * (HANDLE_OUT - r)
    hw = HANDLE_SPAN / 2.0 - r
    R = HANDLE_R
    e = cq.Edge
    V = cq.Vector
    k = math.sqrt(0.5)
    edges = [
        e.makeLine(V(x0, -hw, z), V(xo - direction * R, -hw, z)),
        e.makeThreePointArc(V(xo - direction * R, -hw, z),
                            V(xo - direction * R * (1 - k), -hw + R * (1 - k), z),
                            V(xo, -hw + R, z)),
        e.makeLine(V(xo, -hw + R, z), V(xo, hw - R, z)),
        e.makeThreePointArc(V(xo, hw - R, z),
                            V(xo - direction * R * (1 - k), hw - R * (1 - k), z),
                            V(xo - direction * R, hw, z)),
        e.makeLine(V(xo - direction * R, hw, z), V(x0, hw, z)),
    ]
    path = cq.Wire.assembleEdges(edges)
    prof = cq.Workplane(cq.Plane(origin=(x0, -hw, z), xDir=(0, 0, 1),
                                 normal=(direction, 0, 0))).circle(r)
    return prof.sweep(cq.Workplane(obj=path))


# ---------------- main body: side profile extruded across Y ----------------
profile = [
    (-L / 2 + NX_CH_H, 0.0),
    (L / 2 - PX_CH_H, 0.0),
    (L / 2, PX_CH_V),
    (L / 2, H - SLOPE_DROP),
    (RIDGE_X, H),
    (-L / 2, H),
    (-L / 2, NX_CH_V),
]
body = xz_prism(profile, -W / 2, W / 2)


class _TopSideEdges(cq.Selector):
    """edges where the flat top / slope meet the long side faces"""

    def filter(self, objs):
        out = []
        for e in objs:
            p0, p1 = e.startPoint(), e.endPoint()
            if (abs(abs(p0.y) - W / 2) < 1e-3 and abs(abs(p1.y) - W / 2) < 1e-3
                    and min(p0.z, p1.z) > H - SLOPE_DROP - 1.0
                    and abs(p0.x - p1.x) > 1.0):
                out.append(e)
        return out


TOP_EDGE_R = 4.0
body = body.edges(_TopSideEdges()).fillet(TOP_EDGE_R)

# ---------------- axle bosses (both sides) ----------------
for bx in BOSS_X:
    body = body.union(cyl(BOSS_D / 2, (bx, -W / 2 - BOSS_OUT, BOSS_Z), (0, 1, 0),
                          W + 2 * BOSS_OUT))
    for side in (-1, 1):
        yface = side * (W / 2 + BOSS_OUT)
        body = body.cut(cyl(BOSS_BORE / 2 + 2.0, (bx, yface, BOSS_Z), (0, -side, 0), 4.0))
        body = body.cut(cyl(BOSS_BORE / 2, (bx, yface, BOSS_Z), (0, -side, 0), 26.0))
    # triangular see-through passage along the axle line
    tri = 10.5
    body = body.cut(
        cq.Workplane(mkplane((bx, W / 2 + BOSS_OUT, BOSS_Z), (1, 0, 0), (0, 0, 1)))
        .polyline([(-tri, tri * 0.6), (tri, tri * 0.6), (0, -tri * 1.1)]).close()
        .extrude(W + 2 * BOSS_OUT)
    )

# ---------------- well under the hood ----------------
well = (
    cq.Workplane("XY", origin=(0, 0, WELL_FLOOR_Z))
    .center((HOOD_BACK_X + WELL_END_X) / 2, 0)
    .rect(WELL_END_X - HOOD_BACK_X, HOOD_W - 2 * HOOD_T)
    .extrude(H)
)
body = body.cut(well)

# ---------------- hood: raised flap plate with lip, side walls, back wall ----------------
tip_z = H + HOOD_TIP_RISE
FLAP_X0 = RIDGE_X + 6


def z_flap(x):
    return (H + 1) + (x - FLAP_X0) * (tip_z - (H + 1)) / (HOOD_TIP_X - FLAP_X0)


flap = (
    cq.Workplane(mkplane((0, HOOD_W / 2, 0), (1, 0, 0), (0, 0, 1)))
    .moveTo(FLAP_X0, H + 1)
    .lineTo(HOOD_TIP_X - 4, z_flap(HOOD_TIP_X - 4))
    .threePointArc((HOOD_TIP_X + 0.8, tip_z - 3.0), (HOOD_TIP_X - 1.0, tip_z - 9.0))
    .lineTo(HOOD_TIP_X - 4.0, tip_z - 9.0)
    .threePointArc((HOOD_TIP_X - 2.6, tip_z - 4.5), (HOOD_TIP_X - 5.0, z_flap(HOOD_TIP_X - 5) - HOOD_T))
    .lineTo(FLAP_X0, H + 1 - HOOD_T - 2)
    .close()
    .extrude(HOOD_W)
)


class _FlapTopEdges(cq.Selector):
    """long upper edges of the flap plate (bends into the side walls)"""

    def filter(self, objs):
        out = []
        for e in objs:
            p0, p1 = e.startPoint(), e.endPoint()
            if (abs(abs(p0.y) - HOOD_W / 2) < 1e-3 and abs(abs(p1.y) - HOOD_W / 2) < 1e-3
                    and abs(p0.x - p1.x) > 100
                    and abs(p0.z - z_flap(p0.x)) < 0.05 and abs(p1.z - z_flap(p1.x)) < 0.05):
                out.append(e)
        return out


flap = flap.edges(_FlapTopEdges()).fillet(2.5)


def hood_wall(y0, y1):
    """side wall of the hood: sits on the slope, concave end under the lip"""
    return (
        cq.Workplane(mkplane((0, y1, 0), (1, 0, 0), (0, 0, 1)))
        .moveTo(FLAP_X0 + 1, z_slope(FLAP_X0 + 1) - 2)
        .lineTo(HOOD_END_X, z_slope(HOOD_END_X) - 2)
        .lineTo(HOOD_END_X, H - 6)
        .threePointArc((HOOD_END_X + 18, H - 4.5), (HOOD_TIP_X - 3, tip_z - 8))
        .lineTo(HOOD_TIP_X - 3, z_flap(HOOD_TIP_X - 3) - 1)
        .lineTo(FLAP_X0 + 1, z_flap(FLAP_X0 + 1) - 1)
        .close()
        .extrude(y1 - y0)
    )


hood = flap
for side in (-1, 1):
    y0 = side * HOOD_W / 2 - (HOOD_T if side > 0 else 0)
    hood = hood.union(hood_wall(y0, y0 + HOOD_T))
hood = hood.union(
    xz_prism([(HOOD_BACK_X - HOOD_T, WELL_FLOOR_Z), (HOOD_BACK_X, WELL_FLOOR_Z),
              (HOOD_BACK_X, z_flap(HOOD_BACK_X) - 2),
              (HOOD_BACK_X - HOOD_T, z_flap(HOOD_BACK_X - HOOD_T) - 2)],
             -HOOD_W / 2, HOOD_W / 2)
)
body = body.union(hood)

# D-shaped cut-outs in the chute walls near the floor
cut_back = (
    cq.Workplane(mkplane((HOOD_BACK_X, 0, 0), (0, 1, 0), (0, 0, 1)))
    .center(17, WELL_FLOOR_Z + 25).slot2D(24, 20, 90).extrude(-8)
)
cut_side = (
    cq.Workplane(mkplane((0, HOOD_W / 2 - HOOD_T, 0), (-1, 0, 0), (0, 0, 1)))
    .center(-(HOOD_BACK_X + 20), WELL_FLOOR_Z + 25).slot2D(24, 20, 90).extrude(8)
)
body = body.cut(cut_back).cut(cut_side)

# ---------------- fan grille on the slope ----------------
def arc_slot(wp, rm, w, a0, a1):
    """curved slot (rounded ends) centred on the workplane origin"""
    a0, a1 = math.radians(a0), math.radians(a1)
    am = 0.5 * (a0 + a1)
    ro, ri = rm + w / 2, rm - w / 2

    def p(r, a):
        return (r * math.cos(a), r * math.sin(a))

    def cap(a, sgn):
        c = p(rm, a)
        return (c[0] - sgn * w / 2 * math.sin(a), c[1] + sgn * w / 2 * math.cos(a))

    return (
        wp.moveTo(*p(ro, a0))
        .threePointArc(p(ro, am), p(ro, a1))
        .threePointArc(cap(a1, 1), p(ri, a1))
        .threePointArc(p(ri, am), p(ri, a0))
        .threePointArc(cap(a0, -1), p(ro, a0))
        .close()
    )


fan = slope_wp(FAN_X, FAN_Y)
for i in range(5):
    a = 72 * i
    body = body.cut(arc_slot(fan, FAN_D * 0.44, 3.2, a, a + 50).extrude(-5))
    body = body.cut(arc_slot(fan, FAN_D * 0.31, 3.2, a + 30, a + 75).extrude(-5))
body = body.cut(fan.circle(FAN_D * 0.18).circle(FAN_D * 0.18 - 2.0).extrude(-2))
body = body.cut(fan.circle(FAN_D * 0.07).extrude(-3))
for sx in (-1, 1):
    for sy in (-1, 1):
        body = body.cut(fan.center(sx * FAN_D * 0.44, sy * FAN_D * 0.44)
                        .circle(1.8).extrude(-6))

# two small slots in the flat top
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, H))
    .pushPoints([(-6.0, 55.0), (-6.0, -54.0)])
    .slot2D(16, 5).extrude(-3)
)

# small hole in the slope beside the hood
body = body.cut(slope_wp(119.0, -61.0).circle(2.2).extrude(-6))

# ---------------- small tapered grip block on top (-X, -Y corner) ----------------
BLK_X, BLK_Y = -156.0, -124.5
blk = (
    cq.Workplane("XY", origin=(BLK_X, BLK_Y, H - 1))
    .rect(85, 35).extrude(12, taper=42)
    .faces(">Z").edges().fillet(2.0)
)
body = body.union(blk)

# ---------------- +X end face details ----------------
px = face_wp("x", 1)
px2 = face_wp("x", 1, 2.5)
# raised obround plate
PL_Z = 112.0
body = body.union(px.center(*fpt("x", 1, 0, PL_Z)).slot2D(200, 27).extrude(2.5))
# recessed obround pocket, round ports and screws
body = body.cut(px2.center(*fpt("x", 1, -39, PL_Z)).slot2D(52, 21).extrude(-4))
body = body.cut(px2.pushPoints([fpt("x", 1, y, PL_Z) for y in (19.5, 51)])
                .circle(11).extrude(-1.5))
body = body.cut(px2.pushPoints([fpt("x", 1, y, PL_Z) for y in (-33, 19.5, 51)])
                .circle(8).extrude(-9))
body = body.cut(px2.pushPoints([fpt("x", 1, y, 106) for y in (-83, 81.5)])
                .circle(2.2).extrude(-8))
# round recess upper right and a small hole lower right
body = body.cut(px.center(*fpt("x", 1, 97.5, 152)).circle(17).extrude(-4))
body = body.cut(px.center(*fpt("x", 1, 124, 63)).circle(2.5).extrude(-6))

# ---------------- -X end face details ----------------
nx = face_wp("x", -1)
nx6 = face_wp("x", -1, 6.0)
body = body.cut(nx.center(*fpt("x", -1, 0, 205)).rect(110, 28).extrude(-2.5))
nx_in = face_wp("x", -1, -2.5)
body = body.union(nx_in.pushPoints([fpt("x", -1, y, 205) for y in (-10, 12)])
                  .circle(6).extrude(3.5))
body = body.union(nx_in.center(*fpt("x", -1, 34, 205)).rect(22, 12).extrude(3.0))
body = body.union(nx_in.center(*fpt("x", -1, -36, 203)).rect(18, 8).extrude(2.0))
conn = [(-90, 203), (-127, 197), (90, 196), (-50, 118), (-90, 121), (93, 110)]
for (cy, cz) in conn:
    body = body.union(nx.center(*fpt("x", -1, cy, cz)).circle(8).extrude(6))
    body = body.cut(nx6.center(*fpt("x", -1, cy, cz)).circle(4.5).extrude(-4))

# ---------------- handles on both ends ----------------
body = body.union(handle(L / 2, 1, HANDLE_Z_POS))
body = body.union(handle(-L / 2, -1, HANDLE_Z_NEG))

# ---------------- small round fittings on the long sides ----------------
for side in (-1, 1):
    wp = face_wp("y", side)
    wp2 = face_wp("y", side, 2.0)
    fx, fz = -24.0, 196.0
    body = body.cut(wp.center(*fpt("y", side, fx, fz)).circle(10).extrude(-1.0))
    body = body.cut(wp.center(*fpt("y", side, fx, fz)).circle(7.5).circle(2.5)
                    .extrude(-8))
    body = body.cut(wp.pushPoints([fpt("y", side, fx + dx, fz + dz)
                                   for dx, dz in ((-10, 8), (10, -8))])
                    .circle(1.3).extrude(-4))
    pts = [fpt("y", side, x, 66) for x in (-201, -151, 174, 224)]
    pts += [fpt("y", side, x, 16) for x in (-151, 224)]
    body = body.cut(wp.pushPoints(pts).circle(2.5).extrude(-6))

# ---------------- shallow panel on the underside ----------------
body = body.cut(
    cq.Workplane("XY")
    .center((-127 + 240) / 2, (-78 + 52) / 2)
    .rect(240 + 127, 52 + 78)
    .extrude(1.5)
)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
